import cadquery as cq

# =====================================================================
#  Pedal top cover / lid with humbucker-style window
#  hollow shell, open underneath, internal rebate ledge + skirt,
#  thick back wall with big inside radii (cable notch on the left),
#  front corner screw posts, engraved control legends.
# =====================================================================

# ---------------- overall ----------------
W = 120.0          # overall X
L = 136.0          # overall Y
H = 18.6           # overall Z
R_V = 4.0          # plan-view corner radius
R_TOP = 5.8        # round on the top perimeter edge
T_TOP = 2.2        # top plate thickness
T_WALL = 2.9       # front / side wall thickness above the rebate
T_BACK = 5.5       # back (+Y) wall thickness above the rebate
T_SKIRT = 1.4      # skirt thickness below the rebate
Z_LEDGE = 4.0      # height of the internal rebate ledge

# ---------------- window cut-out ----------------
WIN_CY = 21.1      # window centre (Y)
WIN_W = 83.6       # main rectangle X
WIN_H = 50.0       # main rectangle Y
TAB_W = 108.4      # overall X including the end tabs
TAB_H = 25.0       # tab height (Y)
WIN_R = 4.3        # corner / ear radius

MH_X = 47.4        # small mounting holes beside the window
MH_DY = 17.85
MH_D = 2.0

# ---------------- controls ----------------
KNOB_Y = -53.9
KNOB_PITCH = 17.46
KNOB_D = 6.2
SW_X = 43.3
SW_Y = -28.75
SW_D = 5.4

# ---------------- engraved markings ----------------
ENGR_D = 0.4                        # engraving depth
LABELS = ["Level", "Tone", "Gain", "Jank", "Feedback", "Time"]
LABEL_Y = -40.1
LABEL_SIZE = 3.5
PTR_W = 0.7                         # pointer groove width
PTR_TIP_Y = -43.0                   # pointer end (small dot)
PTR_DOT_D = 1.2
SW_LABELS = [("S", 36.7), ("L", 49.4)]
SW_LABEL_SIZE = 3.2

# ---------------- inside details ----------------
R_BACK = 25.0      # vertical inside radius where the back wall meets the side walls
NOTCH_X0, NOTCH_X1 = -51.6, -48.6   # cable notch cut into the left inside radius
NOTCH_Y1 = 57.0
POST = 8.0         # front corner posts (square)
CORNER_HOLES = [(-54.9, 61.9), (51.9, 61.5), (-55.0, -61.6), (55.0, -61.6)]
CH_D = 4.0
CH_DEPTH = 6.0

# =====================================================================
ZI = H - T_TOP                     # underside of the top plate
IW = W - 2 * T_WALL                # inside width between the side walls

# ---------------- shell ----------------
outer = (cq.Workplane("XY").box(W, L, H, centered=(True, True, False))
         .edges("|Z").fillet(R_V)
         .faces(">Z").edges().fillet(R_TOP))

# cavity above the rebate ledge (thin front/side walls, thick back wall, big back radii)
cav_y0, cav_y1 = -L / 2 + T_WALL, L / 2 - T_BACK
cavity = (cq.Workplane("XY").box(IW, cav_y1 - cav_y0, ZI - Z_LEDGE, centered=(True, False, False))
          .translate((0, cav_y0, Z_LEDGE)))
cavity = cavity.edges("|Z and >Y").fillet(R_BACK)
cavity = cavity.edges("|Z and <Y").fillet(R_V - T_WALL + 0.5)

# rebate under the ledge: thin skirt all round
rebate = (cq.Workplane("XY").box(W - 2 * T_SKIRT, L - 2 * T_SKIRT, Z_LEDGE + 0.02, centered=(True, True, False))
          .edges("|Z").fillet(R_V - T_SKIRT)
          .translate((0, 0, -0.01)))
body = outer.cut(cavity).cut(rebate)

# cable notch cut into the left inside radius of the back wall
notch = (cq.Workplane("XY").box(NOTCH_X1 - NOTCH_X0, 12.0, ZI - Z_LEDGE + 0.5, centered=False)
         .translate((NOTCH_X0, NOTCH_Y1 - 12.0, Z_LEDGE - 0.5)))
body = body.cut(notch)

# ---------------- front corner posts + four screw holes ----------------
for sx in (-1, 1):
    post = (cq.Workplane("XY").box(POST, POST, ZI - Z_LEDGE + 0.2, centered=False)
            .translate((IW / 2 - POST if sx > 0 else -IW / 2, cav_y0, Z_LEDGE)))
    body = body.union(post)
body = body.cut(cq.Workplane("XY").pushPoints(CORNER_HOLES).circle(CH_D / 2)
                .extrude(CH_DEPTH).translate((0, 0, Z_LEDGE - 0.01)))

# ---------------- window through the top plate ----------------
win = (cq.Workplane("XY").rect(WIN_W, WIN_H).extrude(H + 2)
       .union(cq.Workplane("XY").rect(TAB_W, TAB_H).extrude(H + 2))
       .edges("|Z").fillet(WIN_R)
       .translate((0, WIN_CY, -1)))
body = body.cut(win)

# mounting holes around the window
pts = [(sx * MH_X, WIN_CY + sy * MH_DY) for sx in (-1, 1) for sy in (-1, 1)]
body = body.cut(cq.Workplane("XY").pushPoints(pts).circle(MH_D / 2).extrude(H + 2)
                .translate((0, 0, -1)))

# knob holes + switch hole
kpts = [((i - 2.5) * KNOB_PITCH, KNOB_Y) for i in range(6)]
body = body.cut(cq.Workplane("XY").pushPoints(kpts).circle(KNOB_D / 2).extrude(H + 2)
                .translate((0, 0, -1)))
body = body.cut(cq.Workplane("XY").center(SW_X, SW_Y).circle(SW_D / 2).extrude(H + 2)
                .translate((0, 0, -1)))

# ---------------- engraving: labels, pointer grooves, switch legend ----------------
engr = None


def _add(e):
    global engr
    engr = e if engr is None else engr.union(e)


for i, name in enumerate(LABELS):
    kx = (i - 2.5) * KNOB_PITCH
    _add(cq.Workplane("XY").workplane(offset=H).center(kx, LABEL_Y)
         .text(name, LABEL_SIZE, -ENGR_D, kind="regular", halign="center", valign="center", combine=False))
    y0 = KNOB_Y + KNOB_D / 2 - 0.5
    _add(cq.Workplane("XY").workplane(offset=H - ENGR_D)
         .center(kx, (y0 + PTR_TIP_Y) / 2).slot2D(PTR_TIP_Y - y0, PTR_W, angle=90).extrude(ENGR_D + 0.5))
    _add(cq.Workplane("XY").workplane(offset=H - ENGR_D)
         .center(kx, PTR_TIP_Y).circle(PTR_DOT_D / 2).extrude(ENGR_D + 0.5))
for name, sx in SW_LABELS:
    _add(cq.Workplane("XY").workplane(offset=H).center(sx, SW_Y)
         .text(name, SW_LABEL_SIZE, -ENGR_D, kind="regular", halign="center", valign="center", combine=False))
body = body.cut(engr)

result = body
